import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Robot joint module: horizontal drive housing on top, two X-braced side
# plates, lower drive box and bottom output flange.
# Units: mm.  X = housing axis, Z = up, origin at bottom-centre of part.
# ---------------------------------------------------------------------------

# ---- upper housing --------------------------------------------------------
HW = 102.0            # housing square section (Y and Z)
HZC = 306.0           # housing axis height
H_X0 = -124.0         # -X end of end cap
CAP_T = 11.5          # end cap thickness
BODY_X1 = 44.5        # end of main body
RB_S = 11.0           # size of the longitudinal edge rebates of the main body
RB_X0 = -101.5        # rebate start
RB_XE = 39.0          # rebate end
RB_X1 = 67.5          # right block end
EDGE_CH = 4.0         # small chamfer on housing block edges
GB_D = 97.0           # gearbox cylinder diameter
GB_X1 = 101.0         # gearbox end
FL_T = 12.0           # output flange thickness
OUT_RING_D = 92.0
OUT_RING_T = 3.5
OUT_D = 88.0
OUT_T = 8.0

# ---- side plates ----------------------------------------------------------
PL_W = 81.0           # plate width (X)
PL_T = 9.0            # plate thickness (Y)
PL_Z0 = 123.0
PL_Z1 = 345.5
# X-brace cut-outs in the side plates
XC_Z = 201.5          # height of the X crossing
X_HW = 23.5           # half width of the X field
X_TOP = 260.5         # top edge of upper triangle
X_BOT = 142.0         # bottom edge of lower triangle
X_TRI_HW = 15.5       # half width of upper / lower triangles
X_APEX = 23.5         # triangle apex distance from crossing
X_SIDE_H = 27.0       # half height of the side openings
X_SIDE_IN = 10.5      # inner x of side openings (top / bottom corners)
X_SIDE_APEX = 3.0     # side opening apex distance from centre line
X_R = 2.5             # corner rounding of the cut-outs
X_FIL = 2.0           # fillet on the outer edges of the X-brace
CB_R = 5.0            # plate screw counterbore radius
CB_D = 4.0            # plate screw counterbore depth
WIN_D = 4.5           # depth of the window pocket

# ---- lower box -----------------------------------------------------------
LB_W = 101.0          # X
LB_D = 102.0          # Y
LB_Z0 = 56.5
LB_Z1 = 202.5
LB_CH = 4.0
LB_NOTCH = 9.5        # corner notch size
LB_ROD_R = 2.6        # corner tie rod radius
LB_POST_IN = 1.5      # corner posts sit this far below the box faces

# ---- bottom output ----------------------------------------------------------
BC_D = 97.0           # bottom cylinder
GROOVES_Z = (115.6, 99.9, 92.4, 147.5, 156.0, 164.5)   # V-grooves on lower box faces
BF_Z0 = 12.0          # bottom flange
BF_Z1 = 22.5
BF_W = 102.0
BD_D = 98.0           # bottom disc
BD_Z0 = 4.5
BO_D = 78.0           # bottom output disc


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0)
            .translate(((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)))


def cyl(p, d, r, h, seam=0.0):
    s = cq.Solid.makeCylinder(r, h, cq.Vector(*p), cq.Vector(*d))
    if seam:
        s = s.rotate(cq.Vector(*p), cq.Vector(*p) + cq.Vector(*d), seam)
    return cq.Workplane("XY").add(s)


def prism_yz(pts, x0, x1):
    """Polygon in YZ plane (y,z points) extruded along X from x0 to x1."""
    w = cq.Wire.makePolygon([cq.Vector(x0, y, z) for y, z in pts], close=True)
    f = cq.Face.makeFromWires(w)
    s = cq.Solid.extrudeLinear(f, cq.Vector(x1 - x0, 0, 0))
    return cq.Workplane("XY").add(s)


def prism_xz(pts, y0, y1, r=0.0):
    """Polygon in XZ plane (x,z points) extruded from y0 to y1, corners rounded."""
    w = cq.Wire.makePolygon([cq.Vector(x, y0, z) for x, z in pts], close=True)
    if r > 0:
        w = w.offset2D(-r, "arc")[0].offset2D(r, "arc")[0]
    f = cq.Face.makeFromWires(w)
    s = cq.Solid.extrudeLinear(f, cq.Vector(0, y1 - y0, 0))
    return cq.Workplane("XY").add(s)


# ===========================================================================
# Upper housing
# ===========================================================================
h2 = HW / 2
zt, zb = HZC + h2, HZC - h2

cap = (box(H_X0, H_X0 + CAP_T, -h2, h2, zb, zt).edges("|X").chamfer(EDGE_CH)
       .faces("<X").edges("|Z").fillet(3.5))
# main body: square section with rebated longitudinal edges in the middle
body_mid = box(RB_X0, RB_XE, -h2, h2, zb, zt)
for sy in (-1, 1):
    for sz in (-1, 1):
        ya, yb = sy * (h2 - RB_S), sy * (h2 + 1)
        za, zb2 = HZC + sz * (h2 - RB_S), HZC + sz * (h2 + 1)
        body_mid = body_mid.cut(box(RB_X0 - 1, RB_XE + 1,
                                    min(ya, yb), max(ya, yb),
                                    min(za, zb2), max(za, zb2)))
# square portions at both ends of the rebated body
body = (box(H_X0 + CAP_T, RB_X0, -h2, h2, zb, zt).edges("|X").chamfer(EDGE_CH)
        .union(body_mid)
        .union(box(RB_XE, BODY_X1, -h2, h2, zb, zt).edges("|X").chamfer(EDGE_CH)))
rblock = box(BODY_X1, RB_X1, -h2, h2, zb, zt).edges("|X").chamfer(EDGE_CH)
gear = cyl((RB_X1, 0, HZC), (1, 0, 0), GB_D / 2, GB_X1 - RB_X1, seam=180)
oflange = (box(GB_X1, GB_X1 + FL_T, -h2, h2, zb, zt)
           .edges("|X").chamfer(3.0))
oring = cyl((GB_X1 + FL_T, 0, HZC), (1, 0, 0), OUT_RING_D / 2, OUT_RING_T, seam=180)
odisc = cyl((GB_X1 + FL_T + OUT_RING_T, 0, HZC), (1, 0, 0), OUT_D / 2, OUT_T, seam=180)

housing = cap.union(body).union(rblock).union(gear).union(oflange)
housing = housing.union(oring).union(odisc)

# -X end cap ring and bore
capx = H_X0
# shallow annular groove outlining the bearing cover
housing = housing.cut(cyl((capx - 1, 0, HZC), (1, 0, 0), 39.0, 1.8)
                      .cut(cyl((capx - 2, 0, HZC), (1, 0, 0), 37.8, 4.0)))
housing = housing.cut(cyl((capx - 1, 0, HZC), (1, 0, 0), 23.5, 9.0))
for i in range(8):
    a = math.radians(22.5 + 45 * i)
    housing = housing.cut(cyl((capx - 1, 29.0 * math.cos(a), HZC + 29.0 * math.sin(a)),
                              (1, 0, 0), 1.8, 8.0))
for sy in (-1, 1):
    for sz in (-1, 1):
        housing = housing.cut(cyl((capx - 1, sy * 42.0, HZC + sz * 42.0),
                                  (1, 0, 0), 2.6, 8.0))

# output face details
ox = GB_X1 + FL_T + OUT_RING_T + OUT_T
housing = housing.cut(cyl((ox - 4.0, 0, HZC), (1, 0, 0), 23.0, 5.0))
housing = housing.union(cyl((ox - 4.5, 0, HZC), (1, 0, 0), 5.5, 3.5, seam=180))
for i in range(8):
    a = math.radians(45 * i)
    housing = housing.cut(cyl((ox - 6.0, 33.75 * math.cos(a), HZC + 33.75 * math.sin(a)),
                              (1, 0, 0), 2.2, 8.0))
# index mark: narrow radial groove from the top bolt hole to the rim
housing = housing.cut(box(ox - 0.8, ox + 1, -0.6, 0.6, HZC + 33.75, HZC + OUT_D / 2 + 1))
# index mark on the -X end cap
housing = housing.cut(box(capx - 1, capx + 0.8, -0.6, 0.6, HZC + 31.0, HZC + 44.0))
# flange corner holes
for sy in (-1, 1):
    for sz in (-1, 1):
        housing = housing.cut(cyl((GB_X1 - 1, sy * 45.0, HZC + sz * 45.0),
                                  (1, 0, 0), 2.6, FL_T + 2))
# radial holes on flange and right block side faces
for xh in (61.5, GB_X1 + FL_T / 2):
    for s in (-33.5, 33.5):
        housing = housing.cut(cyl((xh, -h2 - 1, HZC + s), (0, 1, 0), 1.8, 8))
        housing = housing.cut(cyl((xh, h2 + 1, HZC + s), (0, -1, 0), 1.8, 8))
        housing = housing.cut(cyl((xh, s, zt + 1), (0, 0, -1), 1.8, 8))
        housing = housing.cut(cyl((xh, s, zb - 1), (0, 0, 1), 1.8, 8))

# side face bolt holes
for xh in (-96.0, -73.0, -50.5):
    for s in (-33.5, 33.5):
        housing = housing.cut(cyl((xh, -h2 - 1, HZC + s), (0, 1, 0), 1.8, 6))
        housing = housing.cut(cyl((xh, h2 + 1, HZC + s), (0, -1, 0), 1.8, 6))
# axial holes in the end walls of the rebates
for sy in (-1, 1):
    for sz in (-1, 1):
        housing = housing.cut(cyl((RB_X0 - 0.01, sy * (h2 - RB_S / 2),
                                   HZC + sz * (h2 - RB_S / 2)), (-1, 0, 0), 2.0, 8))
# top centre hole
housing = housing.cut(cyl((-28.6, 0, zt + 1), (0, 0, -1), 4.5, 4))

# ===========================================================================
# Side plates (front at -Y, back at +Y, identical by mirror)
# ===========================================================================
pw2 = PL_W / 2


def make_plate(sign):
    yo = sign * (h2 + PL_T)      # outer face
    yi = sign * h2               # inner face
    y0, y1 = min(yo, yi), max(yo, yi)
    p = box(-pw2, pw2, y0, y1, PL_Z0, PL_Z1)
    # window pocket on outer face
    wd = WIN_D
    if sign < 0:
        p = p.cut(box(-21.2, 21.2, y0 - 1, y0 + wd, 281.3, 330.0)
                  .edges("|Y").fillet(4.0))
    else:
        p = p.cut(box(-21.2, 21.2, y1 - wd, y1 + 1, 281.3, 330.0)
                  .edges("|Y").fillet(4.0))
    # shallow notch at the bottom edge (clearance for the cable clamp)
    if sign < 0:
        p = p.cut(box(-23.0, 2.3, y0 - 1, y0 + 2.0, PL_Z0 - 1, 136.4))
    else:
        p = p.cut(box(-23.0, 2.3, y1 - 2.0, y1 + 1, PL_Z0 - 1, 136.4))
    # X brace through cut-outs
    zc = XC_Z
    tris = [
        [(-X_TRI_HW, X_TOP), (X_TRI_HW, X_TOP), (0.0, zc + X_APEX)],
        [(-X_TRI_HW, X_BOT), (X_TRI_HW, X_BOT), (0.0, zc - X_APEX)],
    ]
    for sx in (-1, 1):
        tris.append([(sx * X_HW, zc + X_SIDE_H), (sx * X_SIDE_IN, zc + X_SIDE_H),
                     (sx * X_SIDE_APEX, zc), (sx * X_SIDE_IN, zc - X_SIDE_H),
                     (sx * X_HW, zc - X_SIDE_H)])
    for t in tris:
        p = p.cut(prism_xz(t, y0 - 1, y1 + 1, r=X_R))
    # round the outer edges of the X-brace so the ribs read as rounded bars
    p = p.edges(cq.selectors.BoxSelector((-X_HW - 1, yo - 0.2, X_BOT - 3),
                                         (X_HW + 1, yo + 0.2, X_TOP + 3))).fillet(X_FIL)
    # bolt holes with counterbores
    holes = [(x, z) for x in (-28.7, -6.0, 16.5) for z in (338.7, 271.5)]
    holes += [(x, z) for x in (-34.2, 34.2) for z in (174.8, 152.6, 130.4)]
    for x, z in holes:
        p = p.cut(cyl((x, y0 - 1, z), (0, 1, 0), 2.6, PL_T + 2))
        if sign < 0:
            p = p.cut(cyl((x, y0 - 1, z), (0, 1, 0), CB_R, CB_D + 1))
        else:
            p = p.cut(cyl((x, y1 + 1, z), (0, -1, 0), CB_R, CB_D + 1))
    return p


plates = make_plate(-1).union(make_plate(1))

# ===========================================================================
# Lower box
# ===========================================================================
lw2, ld2 = LB_W / 2, LB_D / 2
lbox = box(-lw2, lw2, -ld2, ld2, LB_Z0, LB_Z1).edges("|Z").chamfer(LB_CH)
# vertical corner notches holding tie rods (full blocks at top and bottom)
pz0, pz1 = 70.0, 191.0
for sx in (-1, 1):
    for sy in (-1, 1):
        xa, xb = sx * (lw2 - LB_NOTCH), sx * (lw2 + 1.0)
        ya, yb = sy * (ld2 - LB_NOTCH), sy * (ld2 + 1.0)
        lbox = lbox.cut(box(min(xa, xb), max(xa, xb), min(ya, yb), max(ya, yb), pz0, pz1))
        # corner post sitting slightly below the faces, chamfered like the box edge
        xp, yp = sx * (lw2 - LB_POST_IN), sy * (ld2 - LB_POST_IN)
        post = box(min(xa, xp), max(xa, xp), min(ya, yp), max(ya, yp), pz0 - 1, pz1 + 1)
        post = post.edges("|Z").edges(cq.selectors.NearestToPointSelector(
            (sx * (lw2 + 5), sy * (ld2 + 5), (pz0 + pz1) / 2))).chamfer(LB_CH - 1.0)
        lbox = lbox.union(post)
        # tie rod ends protruding at top and bottom
        rx, ry = sx * (lw2 - LB_NOTCH / 2), sy * (ld2 - LB_NOTCH / 2)
        lbox = lbox.union(cyl((rx, ry, LB_Z1 - 1), (0, 0, 1), LB_ROD_R, 2.5, seam=180))
        lbox = lbox.union(cyl((rx, ry, LB_Z0 + 1), (0, 0, -1), LB_ROD_R, 2.5, seam=180))
# +X face features: slot, hole, rounded pocket
xf = lw2
lbox = lbox.cut(box(xf - 2.0, xf + 1, -23.0, 23.0, 160.8, 174.3).edges("|X").fillet(1.0))
lbox = lbox.cut(cyl((xf + 1, 0, 134.4), (-1, 0, 0), 5.9, 4.0))
lbox = lbox.cut(box(xf - 2.0, xf + 1, -20.7, 20.7, 92.4, 114.9).edges("|X").fillet(5.0))
# -Y / +Y faces below the plates: two grooves + holes
for sy in (-1, 1):
    yf = sy * ld2
    for gzc in GROOVES_Z:
        prof = [(yf + sy * 0.5, gzc - 3.0), (yf + sy * 0.5, gzc + 3.0),
                (yf - sy * 2.5, gzc + 0.8), (yf - sy * 2.5, gzc - 0.8)]
        lbox = lbox.cut(prism_yz(prof, -39.0, 39.0))
    for x in (-33.75, 33.75):
        for z in (107.5, 84.5, 62.4):
            lbox = lbox.cut(cyl((x, yf + sy * 1, z), (0, -sy, 0), 1.8, 6))
# holes near bottom on X faces
for sx in (-1, 1):
    for y in (-33.75, 33.75):
        lbox = lbox.cut(cyl((sx * (lw2 + 1), y, 62.4), (-sx, 0, 0), 1.8, 6))
# ===========================================================================
# Bottom output: cylinder, square flange, discs
# ===========================================================================
bot = cyl((0, 0, BF_Z1), (0, 0, 1), BC_D / 2, LB_Z0 - BF_Z1, seam=180)
bfl = box(-BF_W / 2, BF_W / 2, -BF_W / 2, BF_W / 2, BF_Z0, BF_Z1).edges("|Z").chamfer(4.0)
bot = bot.union(bfl)
bot = bot.union(cyl((0, 0, BD_Z0), (0, 0, 1), BD_D / 2, BF_Z0 - BD_Z0, seam=180))
bot = bot.union(cyl((0, 0, 0), (0, 0, 1), BO_D / 2, BD_Z0, seam=180))
# flange corner holes (vertical) and side holes
for sx in (-1, 1):
    for sy in (-1, 1):
        bot = bot.cut(cyl((sx * 44.0, sy * 44.0, BF_Z1 + 1), (0, 0, -1), 2.2, 13))
for s in (-33.75, 33.75):
    zc = (BF_Z0 + BF_Z1) / 2
    bot = bot.cut(cyl((s, -BF_W / 2 - 1, zc), (0, 1, 0), 1.8, 7))
    bot = bot.cut(cyl((s, BF_W / 2 + 1, zc), (0, -1, 0), 1.8, 7))
    bot = bot.cut(cyl((-BF_W / 2 - 1, s, zc), (1, 0, 0), 1.8, 7))
    bot = bot.cut(cyl((BF_W / 2 + 1, s, zc), (-1, 0, 0), 1.8, 7))
# bottom face: central recess and bolt circle
bot = bot.cut(cyl((0, 0, -1), (0, 0, 1), 24.0, 4.0))
for i in range(16):
    a = math.radians(11.25 + 22.5 * i)
    bot = bot.cut(cyl((31.5 * math.cos(a), 31.5 * math.sin(a), -1), (0, 0, 1), 1.7, 7))

result = housing.union(plates).union(lbox).union(bot)
